import math
import cadquery as cq

# =====================================================================
#  Blended "node" block: a convex, hull-like body that blends
#   - a flat rounded top plate (Z = H),
#   - a flat circular pad on the +X end,
#   - coaxial flat circular pads on the front (-Y) and back (+Y) faces,
#   - a rounded -X end.
#  Units: mm.  X = length, Y = width, Z = height.
# =====================================================================

# ---------------- overall size ----------------
L = 40.0        # length along X
W = 30.2        # width  along Y
H = 35.5        # height along Z

# ---------------- top flat plate ----------------
TOP_X0, TOP_X1 = 17.6, 33.2
TOP_Y0, TOP_Y1 = 4.0, 27.85

# ---------------- +X end pad (disc in the plane X = L) ----------------
DX_YC, DX_ZC, DX_R = 15.45, 22.6, 11.55

# ---------------- front/back pads (discs in Y = 0 and Y = W) ----------
DF_XC, DF_R = 23.4, 12.75
DF_ZC = DF_R                      # pads sit on the floor

# ---------------- small ridges that the +X pad blends into ------------
STOP_X, STOP_Z, STOP_Y0, STOP_Y1 = 39.8, 34.55, 14.3, 16.7     # upper ridge
SBOT_X, SBOT_Z, SBOT_Y0, SBOT_Y1 = 37.9, 7.3, 8.0, 23.0       # lower ridge

# ---------------- rounded -X end ----------------
END_RF, END_RB = 6.25, 5.26       # top-view corner radii of the -X end (front, back)
END_Y0, END_Y1 = 8.58, 23.8       # -X flat strip (top view)
BOT_R = 6.25                      # lower -X corner radius (front view)
SH_R, SH_ZC = 23.88, 12.62        # -X shoulder arc (front view): radius, centre height; centre X = SH_R
SH_END = 107.0                    # deg, where the rolled shoulder edge reaches the top plate
BLEND_END = 135.0                 # deg, how far down the shoulder the plate-corner blend reaches
BLEND_N = 8                       # balls used for the plate-corner blend
END_FILLET = 0.0                  # optional extra blend of the lower -X corners
FRONT_TAPER = 3.9                 # radial growth per mm of depth around the front pad
BACK_TAPER = 3.9                  # same around the back pad

VIEW = {"azimuth": 45, "elevation": 26}

V = cq.Vector


# =====================================================================
#  small geometry helpers
# =====================================================================
def circ_tangent_2d(px, pz, cx, cz, r, sign):
    """tangent point on circle (cx,cz,r) of a line from (px,pz); sign picks the side"""
    dx, dz = px - cx, pz - cz
    d = math.hypot(dx, dz)
    a = math.atan2(dz, dx) + sign * math.acos(r / d)
    return cx + r * math.cos(a), cz + r * math.sin(a), a


def disc_pt(phi_deg):
    a = math.radians(phi_deg)
    return V(L, DX_YC + DX_R * math.cos(a), DX_ZC + DX_R * math.sin(a))


def pad_pt(theta_deg, y):
    a = math.radians(theta_deg)
    return V(DF_XC + DF_R * math.cos(a), y, DF_ZC + DF_R * math.sin(a))


def disc_tangent_normal(p, phi_deg):
    """outward normal of the plane through point p that touches the +X disc at phi"""
    a = math.radians(phi_deg)
    q = disc_pt(phi_deg)
    t = V(0, -math.sin(a), math.cos(a))
    n = (q - p).cross(t)
    n = n.normalized()
    c = V(L, DX_YC, DX_ZC)
    if n.dot(c - q) > 0:
        n = n * -1
    return n


def pad_support(n, y):
    """support value of the front/back pad circle (in plane Y = y) along unit n"""
    c = V(DF_XC, y, DF_ZC)
    return n.dot(c) + DF_R * math.sqrt(max(0.0, 1.0 - n.y * n.y))


def pad_touch_theta(n):
    return math.degrees(math.atan2(n.z, n.x))


def solve(f, lo, hi, steps=200):
    """first sign change of f in [lo, hi], refined by bisection"""
    xs = [lo + (hi - lo) * i / steps for i in range(steps + 1)]
    fs = [f(x) for x in xs]
    for i in range(steps):
        if fs[i] == 0:
            return xs[i]
        if fs[i] * fs[i + 1] < 0:
            a, b, fa = xs[i], xs[i + 1], fs[i]
            for _ in range(60):
                m = 0.5 * (a + b)
                fm = f(m)
                if fa * fm <= 0:
                    b = m
                else:
                    a, fa = m, fm
            return 0.5 * (a + b)
    raise ValueError("no root")


def phi_two_points(p, q, lo, hi):
    """disc angle of the plane through p and q touching the +X disc"""
    return solve(lambda ph: disc_tangent_normal(p, ph).dot(q - p), lo, hi)


def phi_point_pad(p, y, lo, hi):
    """disc angle of the plane through p touching both the +X disc and a pad"""
    ph = solve(lambda ph: pad_support(disc_tangent_normal(p, ph), y)
               - disc_tangent_normal(p, ph).dot(p), lo, hi)
    return ph, pad_touch_theta(disc_tangent_normal(p, ph))


def half_space(n, p, size=300.0):
    """solid {x : n.(x - p) <= 0}"""
    n = n.normalized()
    c = p - n * (size / 2.0)
    xd = n.cross(V(0, 0, 1)) if abs(n.z) < 0.9 else n.cross(V(1, 0, 0))
    pl = cq.Plane(origin=c, xDir=xd, normal=n)
    return cq.Workplane(pl).rect(size, size).extrude(size / 2.0, both=True)


def plane_line_tangent_pad(a, b, y, approx):
    """outward normal of the plane containing line a-b that touches the pad circle in Y=y;
    of the (two) solutions the one closest to the direction 'approx' is returned"""
    d = (b - a).normalized()
    u = d.cross(V(0, 0, 1)) if abs(d.z) < 0.9 else d.cross(V(1, 0, 0))
    u = u.normalized()
    v = d.cross(u).normalized()

    def nrm(t):
        return u * math.cos(t) + v * math.sin(t)

    def f(t):
        return pad_support(nrm(t), y) - nrm(t).dot(a)

    best, n_steps = None, 720
    for i in range(n_steps):
        t0 = 2 * math.pi * i / n_steps
        t1 = 2 * math.pi * (i + 1) / n_steps
        if f(t0) * f(t1) < 0:
            n = nrm(solve(f, t0, t1, 4))
            if best is None or n.dot(approx) > best.dot(approx):
                best = n
    return best


# =====================================================================
#  key points
# =====================================================================
STOP1, STOP2 = V(STOP_X, STOP_Y0, STOP_Z), V(STOP_X, STOP_Y1, STOP_Z)
SBOT1, SBOT2 = V(SBOT_X, SBOT_Y0, SBOT_Z), V(SBOT_X, SBOT_Y1, SBOT_Z)
TOPF = V(TOP_X1, TOP_Y0, H)       # top plate corners seen by the +X pad
TOPB = V(TOP_X1, TOP_Y1, H)


# =====================================================================
#  main body (everything except the +X pad blend)
# =====================================================================
def front_profile():
    """front (X-Z) outline: top plate, upper ridge, round pad, rounded -X end"""
    tx, tz, _ = circ_tangent_2d(STOP_X, STOP_Z, DF_XC, DF_ZC, DF_R, -1)
    a0 = math.atan2(tz - DF_ZC, tx - DF_XC)
    am = 0.5 * (a0 - math.pi / 2)
    mid = (DF_XC + DF_R * math.cos(am), DF_ZC + DF_R * math.sin(am))
    c45 = BOT_R * (1 - math.sqrt(0.5))
    x_top = SH_R - math.sqrt(SH_R ** 2 - (H - SH_ZC) ** 2)
    a_m = 0.5 * math.asin((H - SH_ZC) / SH_R)
    w = (
        cq.Workplane("XZ")
        .moveTo(x_top, H)
        .lineTo(TOP_X1, H)
        .lineTo(STOP_X, STOP_Z)
        .lineTo(tx, tz)
        .threePointArc(mid, (DF_XC, 0.0))
        .lineTo(BOT_R, 0.0)
        .threePointArc((c45, c45), (0.0, BOT_R))
        .lineTo(0.0, SH_ZC)
        .threePointArc((SH_R * (1 - math.cos(a_m)), SH_ZC + SH_R * math.sin(a_m)), (x_top, H))
        .close()
    )
    return w.extrude(-W)            # XZ normal is -Y: extrude towards +Y


def side_profile():
    """side (Y-Z) outline: chamfered top edges"""
    w = (
        cq.Workplane("YZ")
        .moveTo(0.0, 0.0)
        .lineTo(W, 0.0)
        .lineTo(W, 2 * DF_R)
        .lineTo(TOP_Y1, H)
        .lineTo(TOP_Y0, H)
        .lineTo(0.0, 2 * DF_R)
        .close()
    )
    return w.extrude(L)


def top_profile():
    """top (X-Y) outline: rounded -X corners tapering into the pads, +X ridge"""

    def corner(r, cy, py, sgn):
        # tangent from the pad edge point (DF_XC - DF_R, py) to the corner circle
        cx = r
        px = DF_XC - DF_R
        dx, dy = cx - px, cy - py
        dist = math.hypot(dx, dy)
        tdir = math.atan2(dy, dx) + sgn * math.asin(r / dist)
        nrm = tdir + sgn * math.pi / 2
        t = (cx + r * math.cos(nrm), cy + r * math.sin(nrm))
        a = math.atan2(t[1] - cy, t[0] - cx)
        if sgn > 0:
            am = 0.5 * (a - math.pi) if a < 0 else 0.5 * (a + math.pi)
        else:
            am = 0.5 * (a + math.pi) if a > 0 else 0.5 * (a - math.pi)
        m = (cx + r * math.cos(am), cy + r * math.sin(am))
        return t, m

    t0, m0 = corner(END_RF, END_Y0, 0.0, +1)
    t1, m1 = corner(END_RB, END_Y1, W, -1)
    px = DF_XC - DF_R
    w = (
        cq.Workplane("XY")
        .moveTo(px, 0.0)
        .lineTo(DF_XC + DF_R, 0.0)
        .lineTo(STOP_X, STOP_Y0)
        .lineTo(STOP_X, STOP_Y1)
        .lineTo(DF_XC + DF_R, W)
        .lineTo(px, W)
        .lineTo(*t1)
        .threePointArc(m1, (0.0, END_Y1))
        .lineTo(0.0, END_Y0)
        .threePointArc(m0, t0)
        .close()
    )
    return w.extrude(H)


def rounded_end(solid):
    """blend the lower -X corners (where the rounded -X end meets the floor)"""
    edges = []
    for e in solid.Edges():
        bb = e.BoundingBox()
        if e.geomType() == "LINE" or bb.xmax > 4.5 or bb.zmax > BOT_R + 0.5:
            continue
        if bb.ymin < END_Y0 - 1.0 or bb.ymax > END_Y1 + 1.0:
            edges.append(e)
    return solid.fillet(END_FILLET, edges)


def pad_taper(y0, ydir, k):
    """cone around a front/back pad: flat pad at Y=y0, surface recedes outside the pad"""
    depth = W
    return cq.Solid.makeCone(
        DF_R, DF_R + k * depth, depth,
        pnt=V(DF_XC, y0, DF_ZC), dir=V(0, ydir, 0),
    )


body = front_profile().intersect(side_profile()).intersect(top_profile())
if END_FILLET > 0:
    body = cq.Workplane().add(rounded_end(body.val()))



def taper_cone(y_pad_gap, r):
    """cone leaving the pad edge tangent to the rolled shoulder edge (tube radius r whose
    centre line sits y_pad_gap behind the pad).  Returns (radial growth per mm of depth,
    radius (about the shoulder centre) of the line where the cone touches the tube)"""
    rho = SH_R - r
    dr, dy = rho - DF_R, y_pad_gap
    d = math.hypot(dr, dy)
    a = math.atan2(dy, dr) - math.asin(r / d)
    t = dr * math.cos(a) + dy * math.sin(a)
    return 1.0 / math.tan(a), DF_R + t * math.cos(a)


def tritangent_normal(p0, y_pad, y_tube, r, guess):
    """outward normal of the plane through p0 that touches both the pad circle (plane
    Y = y_pad) and the rolled shoulder edge (torus: tube radius r around the shoulder
    centre line in Y = y_tube); damped Newton iteration from 'guess'"""
    c_pad = V(DF_XC, y_pad, DF_ZC)
    c_tor = V(SH_R, y_tube, SH_ZC)
    rho = SH_R - r

    def unit(a, b):
        return V(math.cos(b) * math.cos(a), math.cos(b) * math.sin(a), math.sin(b))

    def f(a, b):
        n = unit(a, b)
        q = math.sqrt(n.x * n.x + n.z * n.z)
        h_pad = n.dot(c_pad) + DF_R * q
        h_tor = n.dot(c_tor) + rho * q + r
        return h_pad - n.dot(p0), h_tor - n.dot(p0)

    g = guess.normalized()
    a, b = math.atan2(g.y, g.x), math.asin(g.z)
    for _ in range(60):
        f1, f2 = f(a, b)
        e = 1e-6
        fa1, fa2 = f(a + e, b)
        fb1, fb2 = f(a, b + e)
        j11, j12 = (fa1 - f1) / e, (fb1 - f1) / e
        j21, j22 = (fa2 - f2) / e, (fb2 - f2) / e
        det = j11 * j22 - j12 * j21
        if abs(det) < 1e-12:
            break
        da = (f1 * j22 - f2 * j12) / det
        db = (j11 * f2 - j21 * f1) / det
        a, b = a - 0.7 * da, b - 0.7 * db
    n = unit(a, b)
    f1, f2 = f(a, b)
    if abs(f1) > 1e-4 or abs(f2) > 1e-4 or n.dot(guess.normalized()) < 0.9:
        return None                       # no such facet: the shoulder edge wraps past the plate
    return n


def shoulder_cutter(y_pad, y_tube, r, front, a_end):
    """material outside the rolled (torus) shoulder edge and its tangent taper cone"""
    big = SH_R + 20.0
    if front:
        y0, y1 = -2.0, y_tube
    else:
        y0, y1 = y_tube, W + 2.0
    a0, a1 = math.radians(180.0), math.radians(a_end)
    pts = [(SH_R, SH_ZC)] + [
        (SH_R + big * math.cos(a0 + (a1 - a0) * i / 4), SH_ZC + big * math.sin(a0 + (a1 - a0) * i / 4))
        for i in range(5)
    ]
    wedge = cq.Workplane("XZ", origin=(0, y0, 0)).polyline(pts).close().extrude(-(y1 - y0))
    # allowed: inside the ring of tube centres, or inside the tube ...
    k, r_touch = taper_cone(abs(y_tube - y_pad), r)
    hole = cq.Solid.makeCylinder(r_touch, y1 - y0 + 2, V(SH_R, y0 - 1, SH_ZC), V(0, 1, 0))
    torus = cq.Solid.makeTorus(SH_R - r, r, V(SH_R, y_tube, SH_ZC), V(0, 1, 0))
    # ... and always inside the taper cone leaving the pad edge
    depth = abs(y_tube - y_pad) + 3.0
    cone = cq.Solid.makeCone(DF_R, DF_R + k * depth, depth,
                             pnt=V(DF_XC, y_pad, DF_ZC), dir=V(0, 1 if front else -1, 0))
    allowed = cq.Workplane().add(hole).union(cq.Workplane().add(torus)).intersect(cq.Workplane().add(cone))
    return wedge.cut(allowed)


def corner_cutter(y_pad, r, front):
    """material outside a spherical lower -X corner of radius r"""
    if front:
        box = cq.Workplane().box(r + 1, y_pad + 1, r + 1, centered=False).translate((-1, -1, -1))
    else:
        box = cq.Workplane().box(r + 1, W + 1 - y_pad, r + 1, centered=False).translate((-1, y_pad, -1))
    return box.cut(cq.Workplane().add(cq.Solid.makeSphere(r, V(r, y_pad, r), angleDegrees1=-90, angleDegrees2=90)))


body = body.cut(shoulder_cutter(0.0, END_Y0, END_RF, True, SH_END))
body = body.cut(shoulder_cutter(W, END_Y1, END_RB, False, SH_END))
body = body.cut(corner_cutter(END_Y0, END_RF, True)).cut(corner_cutter(END_Y1, END_RB, False))

# blend from the top plate's -X corners down onto the rolled shoulder edge:
# hull of the plate corner and balls placed along the rolled edge (cone + ball)
X_TOP = SH_R - math.sqrt(SH_R ** 2 - (H - SH_ZC) ** 2)


def point_ball_hull(p, c, r):
    """convex hull of a point p and a ball (c, r), less the ball: the tangent cone"""
    d = (c - p).Length
    axis = (c - p).normalized()
    half = math.asin(min(0.999, r / d))
    h = d - r * math.sin(half)                       # apex to tangent circle plane
    rc = r * math.cos(half)                          # tangent circle radius
    return cq.Solid.makeCone(0.0, rc, h, pnt=p, dir=axis)   # the ball itself lies in the rolled edge


def corner_blend(y_corner, y_tube, r):
    p0 = V(X_TOP, y_corner, H)
    a_top = math.degrees(math.atan2(H - SH_ZC, X_TOP - SH_R))
    blend = None
    for i in range(BLEND_N):
        a = math.radians(a_top + (BLEND_END - a_top) * i / (BLEND_N - 1))
        c = V(SH_R + (SH_R - r) * math.cos(a), y_tube, SH_ZC + (SH_R - r) * math.sin(a))
        piece = point_ball_hull(p0, c, r)
        blend = piece if blend is None else blend.fuse(piece)
    return blend


vh_ref = front_profile().intersect(side_profile()).intersect(top_profile())
for yc, yt, r in ((TOP_Y0, END_Y0, END_RF), (TOP_Y1, END_Y1, END_RB)):
    body = body.union(vh_ref.intersect(cq.Workplane().add(corner_blend(yc, yt, r))))

# supporting planes around the +X end (top slope, upper corners, sides)
n_top = V(H - STOP_Z, 0, STOP_X - TOP_X1).normalized()
body = body.intersect(half_space(n_top, V(TOP_X1, 0, H)))
n4 = plane_line_tangent_pad(TOPF, STOP1, 0.0, V(0.8, -0.55, 0.25))
n5 = plane_line_tangent_pad(TOPB, STOP2, W, V(0.8, 0.55, 0.25))
n2 = plane_line_tangent_pad(STOP1, SBOT1, 0.0, V(0.97, -0.23, 0.0))
n3 = plane_line_tangent_pad(STOP2, SBOT2, W, V(0.97, 0.23, 0.0))
for n, p in ((n4, TOPF), (n5, TOPB), (n2, STOP1), (n3, STOP2)):
    body = body.intersect(half_space(n, p))

# flat pads on the front and back: the surface recedes around them
def taper_slope(k, gap):
    """never let the pad cone cut into the top plate (gap = plate edge to pad plane)"""
    far = math.hypot(max(TOP_X1 - DF_XC, DF_XC - TOP_X0), H - DF_ZC)
    return max(k, (far - DF_R) / gap * 1.03)


body = body.intersect(cq.Workplane().add(pad_taper(0.0, 1, taper_slope(FRONT_TAPER, TOP_Y0))))
body = body.intersect(cq.Workplane().add(pad_taper(W, -1, taper_slope(BACK_TAPER, W - TOP_Y1))))


# lower ridge blended into the front/back pads (oblique cones) + prism
def loft_to_point(circle_wire, p, normal):
    tip = cq.Wire.makeCircle(0.05, p, normal)
    return cq.Solid.makeLoft([circle_wire, tip], True)


INSET = 0.02     # start the ridge cones just behind the pad faces (keeps the booleans clean)
c1w = cq.Wire.makeCircle(DF_R, V(DF_XC, INSET, DF_ZC), V(0, 1, 0))
c2w = cq.Wire.makeCircle(DF_R, V(DF_XC, W - INSET, DF_ZC), V(0, 1, 0))
k1 = loft_to_point(c1w, SBOT1, V(0, 1, 0))
k2 = loft_to_point(c2w, SBOT2, V(0, 1, 0))
bx, bz, _ = circ_tangent_2d(SBOT_X, SBOT_Z, DF_XC, DF_ZC, DF_R, -1)
ux, uz, _ = circ_tangent_2d(SBOT_X, SBOT_Z, DF_XC, DF_ZC, DF_R, +1)
# wedge between the lower ridge and the floor cylinder (flat band facet, full width)
T0, T1 = V(bx, 0.0, bz), V(bx, W, bz)
A0, A1 = V(DF_XC + 0.2 * DF_R, 0.0, DF_ZC + 0.57 * DF_R), V(DF_XC + 0.2 * DF_R, W, DF_ZC + 0.57 * DF_R)


def poly_face(pts):
    return cq.Face.makeFromWires(cq.Wire.makePolygon(pts, close=True))


wedge = cq.Solid.makeSolid(cq.Shell.makeShell([
    poly_face([T0, SBOT1, SBOT2, T1]),      # band facet
    poly_face([T0, A0, SBOT1]),
    poly_face([T1, SBOT2, A1]),
    poly_face([SBOT1, A0, A1, SBOT2]),
    poly_face([T0, T1, A1, A0]),
])).fix()
body = body.union(cq.Workplane().add(k1)).union(cq.Workplane().add(k2)).union(cq.Workplane().add(wedge))

# =====================================================================
#  +X pad blend: ruled loft from the pad circle to the loop of features
#  it is blended into (ridge ends, top plate corners, front/back pads)
# =====================================================================
phi_a = phi_two_points(STOP1, TOPF, 95, 150)
phi_b, th_a = phi_point_pad(TOPF, 0.0, 140, 200)
phi_c, th_b = phi_point_pad(SBOT1, 0.0, 190, 262)
phi_d, th_d = phi_point_pad(SBOT2, W, 278, 350)
phi_e, th_e = phi_point_pad(TOPB, W, 340, 400)
phi_f = phi_two_points(STOP2, TOPB, 405, 445)
keys = [90.0, phi_a, phi_b, phi_c, 270.0, phi_d, phi_e, phi_f, 450.0]

EPS = 0.4        # deg, width of the tiny arcs that stand for single disc points
dedges = []
for i in range(8):
    a0, a1 = keys[i], keys[i + 1]
    dedges.append(cq.Edge.makeThreePointArc(disc_pt(a0 - EPS), disc_pt(a0), disc_pt(a0 + EPS)))
    dedges.append(cq.Edge.makeThreePointArc(disc_pt(a0 + EPS), disc_pt(0.5 * (a0 + a1)), disc_pt(a1 - EPS)))
wire_disc = cq.Wire.assembleEdges(dedges)

C1A, C1B = pad_pt(th_a, 0.0), pad_pt(th_b, 0.0)
C2A, C2B = pad_pt(th_e, W), pad_pt(th_d, W)
C1M = pad_pt(0.5 * (th_a + th_b), 0.0)
C2M = pad_pt(0.5 * (th_d + th_e), W)
DL = 0.15        # mm, length of the tiny edges that stand for single apex points


def step(p, q):
    return p + (q - p).normalized() * DL


s_stop2, s_stop1 = step(STOP2, STOP1), step(STOP1, TOPF)
s_topf, s_sb1 = step(TOPF, C1A), step(SBOT1, SBOT2)
s_sb2, s_topb = step(SBOT2, C2B), step(TOPB, STOP2)
gedges = [
    cq.Edge.makeLine(s_stop2, STOP1), cq.Edge.makeLine(STOP1, s_stop1),
    cq.Edge.makeLine(s_stop1, TOPF), cq.Edge.makeLine(TOPF, s_topf),
    cq.Edge.makeLine(s_topf, C1A), cq.Edge.makeThreePointArc(C1A, C1M, C1B),
    cq.Edge.makeLine(C1B, SBOT1), cq.Edge.makeLine(SBOT1, s_sb1),
    cq.Edge.makeLine(s_sb1, SBOT2), cq.Edge.makeLine(SBOT2, s_sb2),
    cq.Edge.makeLine(s_sb2, C2B), cq.Edge.makeThreePointArc(C2B, C2M, C2A),
    cq.Edge.makeLine(C2A, TOPB), cq.Edge.makeLine(TOPB, s_topb),
    cq.Edge.makeLine(s_topb, STOP2), cq.Edge.makeLine(STOP2, s_stop2),
]
wire_loop = cq.Wire.assembleEdges(gedges)

# inner planar section buried in the body closes the loft
XIN, SHRINK, YIN, ZIN = 26.0, 0.45, W / 2.0, 18.0
loop_pts = [e.startPoint() for e in gedges]


def inner(p):
    return V(XIN, YIN + SHRINK * (p.y - YIN), ZIN + SHRINK * (p.z - ZIN))


wire_inner = cq.Wire.assembleEdges(
    [cq.Edge.makeLine(inner(loop_pts[i]), inner(loop_pts[(i + 1) % 16])) for i in range(16)]
)
cap = cq.Solid.makeLoft([wire_disc, wire_loop, wire_inner], True)

result = body.union(cq.Workplane().add(cap))
